import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 75.0            # overall width (X)
H = 100.0           # overall height (Z)
R_OUT = 12.0        # plan corner radius of the base plate
T_PLATE = 4.8       # base plate (flange) thickness, back face at +Y
BACK_FILLET = 2.4   # round-over on the back perimeter

MARGIN = 5.3        # flange margin around the raised panel
PW = W - 2 * MARGIN  # raised panel width
PH = H - 2 * MARGIN  # raised panel height
R_PAN = 11.3        # plan corner radius of the raised panel
T_PAN = 4.75        # raised panel height (towards -Y, the front)
PAN_FILLET = 1.8    # round-over on the panel front edge

# side notches cut into the raised panel side walls (4x)
NOTCH_Z0 = 28.3     # distance of notch start from centre (Z)
NOTCH_LEN = 8.7     # notch length along Z
NOTCH_DEPTH_X = 3.5  # how far the notch bites into the side wall
NOTCH_DEPTH_Y = 3.25  # notch height measured from the flange face
NOTCH_OVERSHOOT = 1.5  # cutter runs past the panel side wall

# keyhole pocket on the back face
KH_X = 1.0          # keyhole is slightly off-centre towards +X
KH_D = 13.0         # big circle diameter
KH_SLOT_W = 6.2     # slot width
KH_Z_BOTTOM = 12.0  # bottom of circle above centre
KH_Z_TOP = 32.0     # top of slot above centre
KH_DEPTH = 3.0      # pocket depth

# ---------------- base plate ----------------
# Workplane "XZ": local x = X, local y = Z, normal = -Y
plate = (
    cq.Workplane("XZ")
    .sketch().rect(W, H).vertices().fillet(R_OUT).finalize()
    .extrude(-T_PLATE)          # y from 0 to +T_PLATE (back)
)
plate = plate.faces(">Y").edges().fillet(BACK_FILLET)

# ---------------- raised front panel ----------------
panel = (
    cq.Workplane("XZ")
    .sketch().rect(PW, PH).vertices().fillet(R_PAN).finalize()
    .extrude(T_PAN)             # y from 0 to -T_PAN (front)
)
panel = panel.faces("<Y").edges().fillet(PAN_FILLET)

body = plate.union(panel)

# ---------------- side notches ----------------
cut_w = NOTCH_DEPTH_X + NOTCH_OVERSHOOT
for sx in (-1, 1):
    for sz in (-1, 1):
        cx = sx * (PW / 2 - NOTCH_DEPTH_X + cut_w / 2)
        cz = sz * (NOTCH_Z0 + NOTCH_LEN / 2)
        notch = (
            cq.Workplane("XY")
            .box(cut_w, NOTCH_DEPTH_Y, NOTCH_LEN)
            .translate((cx, -NOTCH_DEPTH_Y / 2, cz))
        )
        body = body.cut(notch)

# ---------------- keyhole pocket on back face ----------------
kh_r = KH_D / 2
kh_cz = KH_Z_BOTTOM + kh_r
slot_top_c = KH_Z_TOP - KH_SLOT_W / 2
kh = (
    cq.Workplane("XZ", origin=(0, T_PLATE, 0))
    .center(KH_X, kh_cz).circle(kh_r).extrude(KH_DEPTH)
)
slot = (
    cq.Workplane("XZ", origin=(0, T_PLATE, 0))
    .center(KH_X, (kh_cz + slot_top_c) / 2)
    .slot2D(slot_top_c - kh_cz + KH_SLOT_W, KH_SLOT_W, angle=90)
    .extrude(KH_DEPTH)
)
body = body.cut(kh).cut(slot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
